import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PL_L = 99.2         # plate length (Y)
PL_W = 66.5         # plate width (X)
PL_CX = 0.15        # plate centre (the dome / pins are placed relative to the
PL_CY = 0.4         #   global origin, the holes relative to the plate centre)
PL_T = 3.7          # plate thickness
PL_R = 15.5         # plate corner radius (plan)
PL_BEV_H = 2.0      # width of the shallow bevel on the top/bottom outer edges
PL_BEV_V = 0.75     # height of that bevel
GAP = 29.4          # clear gap between the two plates

HOLE_D = 17.6       # corner hole diameter
HOLES = [(-22.1, 38.7), (21.3, 38.15), (-21.85, -37.8), (21.65, -37.8)]

# cushion-shaped body under the lower plate: squarish in plan, with an
# elliptical shoulder where it meets the plate and a shallow dome underneath
PIL_CX = 1.6        # small offset of the cushion centre in X
PIL_CY = 0.5        # small offset of the cushion centre in Y
PIL_AX = 31.9       # half-size in X at the widest section
PIL_AY = 33.0       # half-size in Y at the widest section
PIL_KX = 0.75       # X/Y stretch of the roundings (rounded corners are elliptical)
PIL_RC = 31.0       # plan corner radius (before the X stretch)
PIL_H = 23.2        # height below the lower plate
PIL_TOP_R = 16.0    # horizontal reach of the top shoulder (Y direction)
PIL_TOP_V = 8.0     # vertical reach of the top shoulder
PIL_BOT_R = 30.0    # horizontal reach of the bottom dome rounding (Y direction)
PIL_BOT_V = 9.8     # vertical reach of the bottom dome rounding

# square posts joining the plates
POST_A = 2.6
POSTS = [(1.65, -37.4), (-1.3, 37.75)]
POST_UP = 0.6       # protrusion above top plate
POST_DN = 2.6       # protrusion below lower plate

# small square through-holes near the long edges of each plate
SQ_A = 2.2
SQ_HOLES = [(-29.8, 3.9), (28.3, 3.9)]

# loose square pins lying under the part
PIN_W = 2.5         # pin width (X)
PIN_T = 2.6         # pin height (Z)
PIN_F = 0.35        # rounding of the pin's long edges
PIN_C = 0.3         # chamfer round the pin ends
PIN_LIFT = 0.3      # pin underside above the cushion underside
PINS = [  # (x, y_start, y_end)
    (-41.0, -52.6, -13.3),
    (-33.2, -53.6, -13.3),
    (-33.2, -4.8, 33.8),
]


def rounded_outline(z, inset=0.0):
    return (cq.Workplane("XY").workplane(offset=z).center(PL_CX, PL_CY)
            .sketch().rect(PL_W - 2 * inset, PL_L - 2 * inset)
            .vertices().fillet(PL_R - inset).finalize())


def plate(z0):
    ang = math.degrees(math.atan2(PL_BEV_H, PL_BEV_V))
    bot = rounded_outline(z0, PL_BEV_H).extrude(PL_BEV_V, taper=-ang)
    mid = rounded_outline(z0 + PL_BEV_V).extrude(PL_T - 2 * PL_BEV_V)
    top = rounded_outline(z0 + PL_T - PL_BEV_V).extrude(PL_BEV_V, taper=ang)
    p = bot.union(mid).union(top)
    holes = (cq.Workplane("XY").workplane(offset=z0 - 1.0)
             .pushPoints([(PL_CX + hx, PL_CY + hy) for (hx, hy) in HOLES])
             .circle(HOLE_D / 2).extrude(PL_T + 2.0))
    return p.cut(holes)


def scaled(shape, sx, sy, sz):
    """Non-uniform scale of a shape about the origin."""
    m = cq.Matrix([[sx, 0, 0, 0], [0, sy, 0, 0], [0, 0, sz, 0], [0, 0, 0, 1]])
    return shape.transformGeometry(m)


def cushion_half(h, r, top):
    """Rounded block (in un-stretched space) with one rounded end face."""
    blk = (cq.Workplane("XY").workplane(offset=-h)
           .sketch().rect(2 * PIL_AX / PIL_KX, 2 * PIL_AY)
           .vertices().fillet(PIL_RC).finalize()
           .extrude(h))
    return blk.faces(">Z" if top else "<Z").edges().fillet(r).val()


# ---------------- plates ----------------
z_low = 0.0                 # underside of the lower plate
z_top = PL_T + GAP          # underside of the upper plate
lower = plate(z_low)
upper = plate(z_top)

# ---------------- cushion: two rounded halves meeting at the widest section ----
z_split = 0.5 * (PIL_TOP_V + PIL_H - PIL_BOT_V)   # middle of the straight side
s_top = PIL_TOP_V / PIL_TOP_R
s_bot = PIL_BOT_V / PIL_BOT_R
top_half = scaled(cushion_half(z_split / s_top, PIL_TOP_R, True), PIL_KX, 1.0, s_top)
bot_half = scaled(cushion_half((PIL_H - z_split) / s_bot, PIL_BOT_R, False),
                  PIL_KX, 1.0, s_bot)
bot_half = bot_half.translate(cq.Vector(0, 0, -z_split))
pillow = (cq.Workplane("XY").add(top_half).union(cq.Workplane("XY").add(bot_half))
          .translate((PIL_CX, PIL_CY, z_low)))

body = lower.union(upper).union(pillow)

# ---------------- square posts through both plates ----------------
for (x, y) in POSTS:
    post = (cq.Workplane("XY").workplane(offset=z_low - POST_DN)
            .center(x, y).rect(POST_A, POST_A)
            .extrude(2 * PL_T + GAP + POST_DN + POST_UP))
    body = body.union(post)

# small square through-holes near the long edges of both plates
for (x, y) in SQ_HOLES:
    cutter = (cq.Workplane("XY").workplane(offset=z_low - 1.0)
              .center(x, y).rect(SQ_A, SQ_A).extrude(2 * PL_T + GAP + 2.0))
    body = body.cut(cutter)

# ---------------- three loose square pins lying beside the cushion ----------
z_pin = z_low - PIL_H + PIN_LIFT
solids = [body.val()]
for (x, y0, y1) in PINS:
    pin = (cq.Workplane("XY").workplane(offset=z_pin)
           .center(x, (y0 + y1) / 2).rect(PIN_W, abs(y1 - y0)).extrude(PIN_T))
    pin = pin.edges("|Y").fillet(PIN_F)
    pin = pin.faces("<Y or >Y").edges().chamfer(PIN_C)
    solids.append(pin.val())

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])
